import math
import cadquery as cq
import cadquery.func as F

# ---------------- driving dimensions (mm) ----------------
LENGTH = 99.0       # straight extent of the bent sheet (along Y)
WIDTH = 80.0        # extent across the bent profile (along X)
THK = 0.5           # sheet thickness (material lies below the outer surface)
BEND_R = 6.0        # outer bend radius at the two creases

# outer (top) profile in the XZ plane, X measured from the left free edge
TIP_L_Z = 5.95          # height of the left panel circle at X = 0
R_LEFT = 55.9           # radius of the left curved panel
CREASE_L = (27.37, 19.70)   # left crease (curved panel -> land)
LAND_SLOPE = -0.067     # the land between the creases falls slightly to +X
CREASE_R_X = 55.3       # right crease position
TIP_R_Z = 0.0           # height of the right panel circle at X = WIDTH
R_RIGHT = 58.0          # radius of the right curved panel (through crease and (WIDTH, TIP_R_Z))
EDGE_L_X = 0.8          # actual left free edge position on the left circle
EDGE_R_X = 79.2         # actual right free edge position on the right circle
ROT_Z_DEG = 0.75        # the sheet sits turned slightly about Z in the reference frame


# ---------------- derived geometry ----------------
def V(x, z, y=0.0):
    # profile coordinates -> 3D, centred in X
    return cq.Vector(x - WIDTH / 2.0, y, z)


# left panel: circle of radius R_LEFT through (0, TIP_L_Z) and the left crease,
# centre below the sheet
ax, az = 0.0, TIP_L_Z
bx, bz = CREASE_L
mx, mz = (ax + bx) / 2.0, (az + bz) / 2.0
chord = math.hypot(bx - ax, bz - az)
h = math.sqrt(R_LEFT ** 2 - (chord / 2.0) ** 2)
ux, uz = (bz - az) / chord, -(bx - ax) / chord      # unit normal pointing down
cxl, czl = mx + ux * h, mz + uz * h

crease_r = (CREASE_R_X, CREASE_L[1] + LAND_SLOPE * (CREASE_R_X - CREASE_L[0]))
tip_r = (WIDTH, TIP_R_Z)

# right panel: circle of radius R_RIGHT through the right crease and
# (WIDTH, TIP_R_Z), centre below the sheet
px, pz = crease_r
qx, qz = tip_r
chord_r = math.hypot(qx - px, qz - pz)
h_r = math.sqrt(R_RIGHT ** 2 - (chord_r / 2.0) ** 2)
vx, vz = (qz - pz) / chord_r, -(qx - px) / chord_r
if vz > 0:
    vx, vz = -vx, -vz
cxr, czr = (px + qx) / 2.0 + vx * h_r, (pz + qz) / 2.0 + vz * h_r

# free edges of the sheet, on the two panel circles
def on_circle_up(cx, cz, r, x):
    return (x, cz + math.sqrt(r * r - (x - cx) ** 2))

edge_l = on_circle_up(cxl, czl, R_LEFT, EDGE_L_X)
edge_r = on_circle_up(cxr, czr, R_RIGHT, EDGE_R_X)
mid_l = on_circle_up(cxl, czl, R_LEFT, 0.5 * (EDGE_L_X + bx))
mid_r = on_circle_up(cxr, czr, R_RIGHT, 0.5 * (crease_r[0] + EDGE_R_X))

# ---------------- outer surface (open profile swept along Y) ----------------
e_left = cq.Edge.makeThreePointArc(V(*edge_l), V(*mid_l), V(bx, bz))
e_land = cq.Edge.makeLine(V(bx, bz), V(*crease_r))
e_right = cq.Edge.makeThreePointArc(V(*crease_r), V(*mid_r), V(*edge_r))
profile = cq.Wire.assembleEdges([e_left, e_land, e_right])

skin = F.extrude(profile, (0, LENGTH, 0))


def nearest_edge(shape, pt):
    return min(shape.Edges(), key=lambda e: (e.Center() - pt).Length)


# soften the creases with a bend radius, then give the skin its thickness
creases = F.compound([
    nearest_edge(skin, V(bx, bz, LENGTH / 2.0)),
    nearest_edge(skin, V(crease_r[0], crease_r[1], LENGTH / 2.0)),
])
skin = F.fillet(skin, creases, BEND_R)
sheet = F.offset(skin, THK)          # thicken towards the concave (under) side
if sheet.BoundingBox().zmax > skin.BoundingBox().zmax + 0.5 * THK:
    sheet = F.offset(skin, -THK)     # (guard against a flipped skin normal)

sheet = sheet.translate(cq.Vector(0, -LENGTH / 2.0, 0))
sheet = sheet.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ROT_Z_DEG)

result = cq.Workplane("XY").add(sheet)

VIEW = {"azimuth": 45, "elevation": 26}
